import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # enclosure length (X)
W = 81.0           # enclosure width  (Y)
HB = 56.7          # body height
HL = 9.6           # lid height
RV = 3.8           # plan corner radius (vertical edges)
RB_BOT = 3.6       # body bottom edge fillet
RB_TOP = 3.3       # body top edge fillet
RL_TOP = 3.7       # lid top edge fillet
RL_BOT = 3.6       # lid bottom edge fillet
WALL = 5.0         # wall / floor thickness of the body

# lid screw holes
HOLE_INSET = 7.1   # hole centre distance from the outer edges
HOLE_D = 5.0
BOSS_R = 5.0       # internal screw boss radius
PILOT_D = 0.0

# shallow label recess on the lid (insets from lid edges)
REC_LEFT, REC_RIGHT, REC_FRONT, REC_BACK = 4.4, 8.4, 5.2, 7.2
REC_DEPTH = 0.5

# cable openings
OPX_W, OPX_Z0, OPX_Z1 = 22.8, 6.3, 16.2     # +X face opening (Y width, z range)
OMX_W, OMX_Z0, OMX_Z1 = 12.9, 41.8, 48.4    # -X face opening
OP_R = 0.0

# loose screws standing beside the box
SCREW_LEN = 31.4
SCREW_SHANK_D = 4.8
SCREW_HEAD_D = 8.0
SCREW_NECK_R = 6.0
SCREW_TIP_D = 1.6
SCREW_CONE_D = 4.5
SCREW_CONE_H = 1.75
SCREW_XS = (86.2, 99.3)
SCREW_YS = (22.7, 32.5)

hx = L / 2 - HOLE_INSET
hy = W / 2 - HOLE_INSET
hole_pts = [(sx * hx, sy * hy) for sx in (-1, 1) for sy in (-1, 1)]

# ---------------- body ----------------
outer = (
    cq.Workplane("XY")
    .sketch().rect(L, W).vertices().fillet(RV).finalize()
    .extrude(HB)
)
outer = outer.faces("<Z").edges().fillet(RB_BOT)
outer = outer.faces(">Z").edges().fillet(RB_TOP)

cavity = (
    cq.Workplane("XY").workplane(offset=WALL)
    .sketch().rect(L - 2 * WALL, W - 2 * WALL).vertices().fillet(1.0).finalize()
    .extrude(HB)
)
bosses = (
    cq.Workplane("XY").workplane(offset=WALL - 0.1)
    .pushPoints(hole_pts).circle(BOSS_R).extrude(HB - WALL + 0.1)
)
cavity = cavity.cut(bosses)
body = outer.cut(cavity)

# pilot holes in the bosses (optional; 0 disables)
if PILOT_D > 0:
    body = body.cut(
        cq.Workplane("XY").workplane(offset=HB - 20.0)
        .pushPoints(hole_pts).circle(PILOT_D / 2).extrude(21.0)
    )

# opening in +X wall (near the bottom)
def wall_opening(x0, width, z0, z1, depth):
    wp = (
        cq.Workplane("YZ").workplane(offset=x0)
        .center(0, (z0 + z1) / 2)
    )
    if OP_R > 0:
        return wp.sketch().rect(width, z1 - z0).vertices().fillet(OP_R).finalize().extrude(depth)
    return wp.rect(width, z1 - z0).extrude(depth)


opx = wall_opening(L / 2 - WALL - 1.0, OPX_W, OPX_Z0, OPX_Z1, WALL + 3.0)
# opening in -X wall (near the top)
omx = wall_opening(-L / 2 - 2.0, OMX_W, OMX_Z0, OMX_Z1, WALL + 3.0)
body = body.cut(opx).cut(omx)

# ---------------- lid ----------------
lid = (
    cq.Workplane("XY").workplane(offset=HB)
    .sketch().rect(L, W).vertices().fillet(RV).finalize()
    .extrude(HL)
)
lid = lid.faces(">Z").edges().fillet(RL_TOP)
lid = lid.faces("<Z").edges().fillet(RL_BOT)

rec_w = L - REC_LEFT - REC_RIGHT
rec_h = W - REC_FRONT - REC_BACK
rec_cx = (-L / 2 + REC_LEFT + L / 2 - REC_RIGHT) / 2
rec_cy = (-W / 2 + REC_FRONT + W / 2 - REC_BACK) / 2
recess = (
    cq.Workplane("XY").workplane(offset=HB + HL - REC_DEPTH)
    .center(rec_cx, rec_cy).rect(rec_w, rec_h).extrude(REC_DEPTH + 1.0)
)
lid = lid.cut(recess)
lid = lid.cut(
    cq.Workplane("XY").workplane(offset=HB - 1.0)
    .pushPoints(hole_pts).circle(HOLE_D / 2).extrude(HL + 2.0)
)

# ---------------- screws ----------------
def make_screw():
    rs = SCREW_SHANK_D / 2
    R = SCREW_HEAD_D / 2
    rf = SCREW_NECK_R
    zc = SCREW_LEN - R                       # head sphere centre
    dz = math.sqrt((R + rf) ** 2 - (rs + rf) ** 2)
    zf = zc - dz                             # neck fillet centre height
    # tangent point on the sphere
    vx, vz = (rs + rf), (zf - zc)
    n = math.hypot(vx, vz)
    px, pz = R * vx / n, zc + R * vz / n
    # mid point on the concave neck arc
    a0 = math.atan2(0.0, -1.0)               # towards shank (pointing -x from fillet centre)
    a1 = math.atan2(pz - zf, px - (rs + rf))
    am = (a0 + a1) / 2
    mx, mz = (rs + rf) + rf * math.cos(am), zf + rf * math.sin(am)
    tip_r = SCREW_TIP_D / 2
    cone_r = SCREW_CONE_D / 2
    cone_h = SCREW_CONE_H
    prof = (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(tip_r, 0)
        .lineTo(cone_r, cone_h)
        .lineTo(rs, cone_h)
        .lineTo(rs, zf)
        .threePointArc((mx, mz), (px, pz))
        .threePointArc((R, zc), (0, zc + R))
        .close()
    )
    return prof.revolve(360, (0, 0, 0), (0, 1, 0))


screw_proto = make_screw()
screws = []
for sx in SCREW_XS:
    for sy in SCREW_YS:
        screws.append(screw_proto.translate((sx, sy, 0)))

parts = [body.val(), lid.val()] + [s.val() for s in screws]
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(parts)])

VIEW = {"azimuth": 45, "elevation": 26}
